"""Eye bracket: a flat plate with a large eye hole on a round end and a
rectangular arm carrying, on its back face, a filleted mounting block with a
tilted through hole, a counterbored web around a second hole and a cylindrical
boss with a blind hole.  Front face of the plate at Y=0, back structure toward +Y.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
T = 5.5            # plate thickness (front face at Y=0, back face at Y=T)
R_OUT = 30.8       # outer radius of the round eye end
HOLE_D = 40.3      # big eye hole diameter
Z_TOP = 21.4       # top edge of the rectangular arm
Z_BOT = -39.3      # bottom edge of the rectangular arm
X_RU = 64.1        # right edge, upper part
X_RL = 58.7        # right edge, lower part
Z_STEP_LO = -3.0   # start of the right-edge step (lower)
Z_STEP_HI = 4.1    # end of the right-edge step (upper)
R_TR = 4.3         # top-right corner radius
R_BR = 2.1         # bottom-right corner radius
X_NECK_TOP = 31.5  # where the upper S-shaped neck meets the top edge
X_NECK_BOT = 35.5  # where the lower S-shaped neck meets the bottom edge

# holes in the plate
UH_X, UH_Z, UH_D, UH_TILT = 45.2, 10.7, 8.9, 27.0   # upper, tilted hole
LH_X, LH_Z, LH_D = 48.9, -9.9, 6.5                  # lower straight hole

# back structure
OFFS = 1.95            # top / +X outline of the back structure = plate outline offset inward
BLK_X0 = 39.3          # -X face of the block
BLK_X1 = X_RU - OFFS   # +X face of the block
BLK_Z0 = 1.7           # underside of the deep block
BLK_Z1 = Z_TOP - OFFS  # top of the block
Y_BLK = 16.3           # back face of block (from plate front)
Y_MID = 12.4           # back face of middle web
Y_BOSS = 18.2          # end face of boss
WEB_X0 = 42.2          # -X wall of the web below the block
LOBE_R = X_RL - OFFS - LH_X   # web lobe around the lower hole (tangent to the offset +X wall)
SL_Z0, SL_Z1 = -3.5, 3.5   # Z span of the -X side S-step (block face -> web wall)
WAIST_X0, WAIST_X1 = 45.4, 53.3   # narrow neck between lobe and boss
CB_D = 11.7            # counterbore in web, coaxial with lower hole
BOSS_X, BOSS_Z = LH_X, -29.4   # boss coaxial (in X) with the lower hole
BOSS_D = 12.3
BOSS_HOLE_D = 4.9
BOSS_HOLE_DEPTH = 9.0
CORNER_R = 2.0         # rounding of the block top -X corner (edges along Y)
WAIST_R = 3.0          # waist-to-boss rounding
LOBE_WAIST_R = 8.0     # lobe-to-waist rounding
WEB_R = 1.9            # web-to-lobe concave rounding
BLK_BOT_R = 2.0        # lower +X corner of the deep block
BASE_FILLET = 1.8      # fillet where the back structure meets the plate
BLK_CHAMFER = 1.8      # block underside to web transition
BOSS_FILLET = 1.5      # boss to web transition

VIEW = {"azimuth": 45, "elevation": 26}


def xz(y=0.0):
    """Workplane parallel to XZ whose extrude goes toward +Y starting at Y=y."""
    return cq.Workplane(cq.Plane(origin=(0, y, 0), xDir=(1, 0, 0), normal=(0, 1, 0)))


# with normal +Y, local x = X but local y = -Z
def P(x, z):
    return (x, -z)


# 3D helpers for faces lying in the plane Y = y
def V3(x, z, y=T):
    return cq.Vector(x, y, z)


def line(a, b, y=T):
    return cq.Edge.makeLine(V3(*a, y), V3(*b, y))


def spl(a, b, ta, tb, y=T):
    return cq.Edge.makeSpline([V3(*a, y), V3(*b, y)],
                              tangents=[cq.Vector(ta[0], 0, ta[1]), cq.Vector(tb[0], 0, tb[1])])


def face_of(edges):
    f = cq.Face.makeFromWires(cq.Wire.assembleEdges(edges))
    if f.normalAt().y < 0:
        f = cq.Face(f.wrapped.Reversed())
    return f


def rect_face(x0, z0, x1, z1, y=T):
    return face_of([line((x0, z0), (x1, z0), y), line((x1, z0), (x1, z1), y),
                    line((x1, z1), (x0, z1), y), line((x0, z1), (x0, z0), y)])


def circle_face(x, z, r, y=T):
    e = cq.Edge.makeCircle(r, V3(x, z, y), cq.Vector(0, 1, 0))
    return face_of([e])


def pick_vertices(face, pts, tol=0.05):
    out = []
    for v in face.Vertices():
        for (x, z) in pts:
            if abs(v.X - x) < tol and abs(v.Z - z) < tol:
                out.append(v)
                break
    return out


def ycyl(x, z, r, y0, h, seam_deg=0.0):
    """Cylinder along +Y (axis through X=x, Z=z) from Y=y0, seam placed at seam_deg in XZ."""
    a = math.radians(seam_deg)
    pl = cq.Plane(origin=(x, y0, z), xDir=(math.cos(a), 0, math.sin(a)), normal=(0, 1, 0))
    return cq.Workplane(pl).circle(r).extrude(h)


def prism(face, depth):
    return cq.Solid.extrudeLinear(face, cq.Vector(0, depth, 0))


# ---------------- plate outline ----------------
s45 = math.sqrt(0.5)

prof = (
    xz(0)
    .moveTo(*P(0.0, R_OUT))
    .threePointArc(P(-R_OUT, 0.0), P(0.0, -R_OUT))
    .spline([P(X_NECK_BOT, Z_BOT)], tangents=[(1, 0), (1, 0)], includeCurrent=True)
    .lineTo(*P(X_RL - R_BR, Z_BOT))
    .threePointArc(P(X_RL - R_BR + R_BR * s45, Z_BOT + R_BR - R_BR * s45), P(X_RL, Z_BOT + R_BR))
    .lineTo(*P(X_RL, Z_STEP_LO))
    .spline([P(X_RU, Z_STEP_HI)], tangents=[(0, -1), (0, -1)], includeCurrent=True)
    .lineTo(*P(X_RU, Z_TOP - R_TR))
    .threePointArc(P(X_RU - R_TR + R_TR * s45, Z_TOP - R_TR + R_TR * s45), P(X_RU - R_TR, Z_TOP))
    .lineTo(*P(X_NECK_TOP, Z_TOP))
    .spline([P(0.0, R_OUT)], tangents=[(-1, 0), (-1, 0)], includeCurrent=True)
    .close()
)
plate = prof.extrude(T)
plate = plate.cut(ycyl(0, 0, HOLE_D / 2, -1, T + 2, 90))

# ---------------- back structure footprint (2D, in plane Y=T) ----------------
LX, LZ = LH_X, LH_Z
web_x1 = LX + LOBE_R                                     # +X wall tangent to the lobe
za = LZ + math.sqrt(LOBE_R ** 2 - (LX - WEB_X0) ** 2)     # -X wall meets lobe here
am_ = math.radians(255.0)
z_in = BLK_Z1 - 6.0                                      # overlap into the block

# +X side S-step of the back structure: the plate's S-step offset inward by OFFS
_step = cq.Edge.makeSpline([cq.Vector(X_RL, 0, Z_STEP_LO), cq.Vector(X_RU, 0, Z_STEP_HI)],
                           tangents=[cq.Vector(0, 0, 1), cq.Vector(0, 0, 1)])
_off_pts = []
for _t in (0.0, 0.25, 0.5, 0.75, 1.0):
    _p = _step.positionAt(_t)
    _d = _step.tangentAt(_t)
    _off_pts.append(V3(_p.x - OFFS * _d.z, _p.z + OFFS * _d.x))
step_off = cq.Edge.makeSpline(_off_pts, tangents=[cq.Vector(0, 0, 1), cq.Vector(0, 0, 1)])
f_web = face_of([
    line((BLK_X0, z_in), (BLK_X0, SL_Z1)),
    spl((BLK_X0, SL_Z1), (WEB_X0, SL_Z0), (0, -1), (0, -1)),
    line((WEB_X0, SL_Z0), (WEB_X0, za)),
    cq.Edge.makeThreePointArc(V3(WEB_X0, za), V3(LX + LOBE_R * math.cos(am_), LZ + LOBE_R * math.sin(am_)),
                              V3(web_x1, LZ)),
    line((web_x1, LZ), (web_x1, Z_STEP_LO)),
    step_off,
    line((BLK_X1, Z_STEP_HI), (BLK_X1, z_in)),
    line((BLK_X1, z_in), (BLK_X0, z_in)),
])
f_top = rect_face(BLK_X0, z_in - 1.0, BLK_X1, BLK_Z1)
f_waist = rect_face(WAIST_X0, BOSS_Z, WAIST_X1, LZ - 2.0)
f_boss = circle_face(BOSS_X, BOSS_Z, BOSS_D / 2)

foot = f_top.fuse(f_web).fuse(f_waist).fuse(f_boss).clean().Faces()[0]


def circ_z(cx_, cz_, r_, x_, sign):
    return cz_ + sign * math.sqrt(r_ ** 2 - (x_ - cx_) ** 2)


zb_l = circ_z(BOSS_X, BOSS_Z, BOSS_D / 2, WAIST_X0, 1)
zb_r = circ_z(BOSS_X, BOSS_Z, BOSS_D / 2, WAIST_X1, 1)
zl_l = circ_z(LX, LZ, LOBE_R, WAIST_X0, -1)
zl_r = circ_z(LX, LZ, LOBE_R, WAIST_X1, -1)
foot = foot.fillet2D(CORNER_R, pick_vertices(foot, [(BLK_X0, BLK_Z1)]))
foot = foot.fillet2D(R_TR - OFFS, pick_vertices(foot, [(BLK_X1, BLK_Z1)]))
foot = foot.fillet2D(WEB_R, pick_vertices(foot, [(WEB_X0, za)]))
foot = foot.fillet2D(LOBE_WAIST_R, pick_vertices(foot, [(WAIST_X0, zl_l), (WAIST_X1, zl_r)]))
foot = foot.fillet2D(WAIST_R, pick_vertices(foot, [(WAIST_X0, zb_l), (WAIST_X1, zb_r)]))

# the deeper block = the footprint above the block underside
blk_face = foot.intersect(rect_face(BLK_X0 - 1, BLK_Z0, BLK_X1 + 1, BLK_Z1 + 1)).Faces()[0]
blk_face = blk_face.translate(cq.Vector(0, Y_MID - T, 0))
blk = cq.Workplane().add(prism(blk_face, Y_BLK - Y_MID))
# round the lower +X corner of the deep block (edge running along Y)
blk = blk.edges("|Y").edges(cq.selectors.BoxSelector(((BLK_X0 + BLK_X1) / 2, Y_MID - 1, BLK_Z0 - 0.01),
                                                      (BLK_X1 + 1, Y_BLK + 1, BLK_Z0 + 0.01))).fillet(BLK_BOT_R)

back = (
    cq.Workplane().add(prism(foot, Y_MID - T))
    .union(blk)
    .union(ycyl(BOSS_X, BOSS_Z, BOSS_D / 2, T, Y_BOSS - T, 230))
    .clean()
)

# 45 deg chamfer-like transition under the block, trimmed to the footprint
c = BLK_CHAMFER
wedge = (
    cq.Workplane("YZ", origin=(BLK_X0 - 1.0, 0, 0))
    .polyline([(Y_MID - 0.3, BLK_Z0 + 0.3), (Y_MID + c, BLK_Z0 + 0.3), (Y_MID + c, BLK_Z0),
               (Y_MID, BLK_Z0 - c), (Y_MID - 0.3, BLK_Z0 - c)])
    .close()
    .extrude(BLK_X1 - BLK_X0 + 2.0)
)
foot_tall = cq.Workplane().add(prism(foot, Y_BLK - T))
wedge = wedge.intersect(foot_tall)

# concave fillet ring where the boss rises from the web: a revolved quarter-round
# profile around the boss axis (seam placed on the hidden lower-left side),
# trimmed to the footprint so it only exists where the web surrounds the boss
rf = BOSS_FILLET
rb = BOSS_D / 2
a_s = math.radians(230)
ring_plane = cq.Plane(origin=(BOSS_X, Y_MID, BOSS_Z), xDir=(math.cos(a_s), 0, math.sin(a_s)),
                      normal=(-math.sin(a_s), 0, math.cos(a_s)))
ring = (
    cq.Workplane(ring_plane)
    .moveTo(rb, 0)
    .lineTo(rb + rf, 0)
    .threePointArc((rb + rf - rf * s45, rf - rf * s45), (rb, rf))
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .intersect(cq.Workplane().add(prism(foot, Y_MID + rf - T)))
)

back = back.union(ring).union(wedge)

part = plate.union(back)

# fillet where the back structure meets the plate (edges of the footprint outline on Y=T)
outline = foot.outerWire()


def _base_edge(e):
    bb = e.BoundingBox()
    if abs(bb.ymin - T) > 1e-3 or abs(bb.ymax - T) > 1e-3:
        return False
    p = e.positionAt(0.5)
    return outline.distance(cq.Vertex.makeVertex(p.x, p.y, p.z)) < 1e-3


part = part.newObject([e for e in part.edges().vals() if _base_edge(e)]).fillet(BASE_FILLET)

# ---------------- holes ----------------
# lower straight hole through the plate
part = part.cut(xz(-1).center(*P(LH_X, LH_Z)).circle(LH_D / 2).extrude(T + 2))
# counterbore through the web down to the plate back face (coaxial with lower hole)
part = part.cut(ycyl(LH_X, LH_Z, CB_D / 2, T, Y_BLK, 230))
# blind hole in the boss
part = part.cut(ycyl(BOSS_X, BOSS_Z, BOSS_HOLE_D / 2, Y_BOSS - BOSS_HOLE_DEPTH, BOSS_HOLE_DEPTH + 1, 230))
# upper hole, tilted in the XY plane, through plate and block
tilt = math.radians(UH_TILT)
axis = cq.Vector(math.sin(tilt), math.cos(tilt), 0)
start = cq.Vector(UH_X, 0, UH_Z) - axis * 20
uh_plane = cq.Plane(origin=start.toTuple(), xDir=(0, 0, 1), normal=axis.toTuple())   # seam on top
part = part.cut(cq.Workplane(uh_plane).circle(UH_D / 2).extrude(60.0))

result = part
